import cadquery as cq

# ---------------------------------------------------------------
# Rounded rectangular block (pad / cover blank)
# Driving dimensions (mm)
# ---------------------------------------------------------------
LENGTH_X = 50.0   # width along X
LENGTH_Y = 70.0   # depth along Y
HEIGHT_Z = 13.0   # thickness along Z
CORNER_R = 2.75   # radius of the four vertical corner edges
EDGE_R = 0.8      # fillet on the top and bottom perimeter edges

# Base block: rounded-rectangle profile extruded along Z, centred on origin
result = (
    cq.Workplane("XY")
    .workplane(offset=-HEIGHT_Z / 2.0)
    .sketch()
    .rect(LENGTH_X, LENGTH_Y)
    .vertices()
    .fillet(CORNER_R)
    .finalize()
    .extrude(HEIGHT_Z)
)

# Soften top and bottom perimeter edges
result = result.faces(">Z or <Z").edges().fillet(EDGE_R)

VIEW = {"azimuth": 45, "elevation": 26}
